"""Pipe-clamp half (saddle clamp) with tilted bolting feet.

Bore axis along Y, part symmetric about the YZ plane.  The split faces of the
clamp (the foot bottoms) are planes tilted by THETA and offset slightly from
the bore axis; each foot is a rectangular block in that tilted frame with a
bolt hole normal to it.  The arch is a flatter, non-concentric outer arc.
The front face carries a shallow counterbore; the back face has small edge
chamfers, the foot ends a front fillet and a back chamfer.
"""
import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
R_BORE = 29.9          # main bore radius (back portion)
R_CBORE = 33.0         # counterbore radius (front portion)
CBORE_DEPTH = 6.0      # counterbore depth from the front face
DEPTH = 18.5           # part depth along Y (bore axis)

R_OUT = 86.75          # outer arch radius
OUT_CZ = -47.8         # outer arch centre height (below the bore axis)

THETA = 11.4           # tilt of the split / foot faces (deg)
FOOT_V_BOT = 2.2       # offset of the foot bottom plane from the bore axis
FOOT_V_TOP = 20.53     # offset of the foot top plane from the bore axis
FOOT_END = 60.7        # distance of the foot end face from the axis (along foot)

HOLE_U = 52.9          # bolt-hole position along the foot
HOLE_D = 7.0           # bolt-hole diameter

END_FILLET = 3.5       # fillet on the front vertical edges of the foot ends
END_CHAMFER = 3.2      # chamfer on the back vertical edges of the foot ends
EDGE_CHAMFER = 0.8     # small chamfer round the back face
BORE_FILLET = 1.5      # fillet where the bore meets the foot bottoms

# ---------------- derived geometry ----------------
th = math.radians(THETA)
s, c = math.sin(th), math.cos(th)
YF, YB = -DEPTH / 2.0, DEPTH / 2.0


def foot_pt(u, v, side):
    """XZ point from foot-frame coords: u along the foot, v normal to it.
    side = -1 for the left (-X) foot, +1 for the right (+X) foot."""
    x = -u * c + v * s
    z = u * s + v * c
    return (x if side < 0 else -x, z)


def outer_top_intersection():
    """Left foot top plane (x*s + z*c = V_TOP) meets the outer arch circle."""
    f = lambda x: x * x + ((FOOT_V_TOP - x * s) / c - OUT_CZ) ** 2 - R_OUT ** 2
    lo, hi = -R_OUT, 0.0
    for _ in range(200):
        mid = 0.5 * (lo + hi)
        if f(lo) * f(mid) <= 0:
            hi = mid
        else:
            lo = mid
    x = 0.5 * (lo + hi)
    return (x, (FOOT_V_TOP - x * s) / c)


p1 = outer_top_intersection()                                             # left top-inner
p8 = foot_pt(FOOT_END, FOOT_V_TOP, -1)                                    # left top-outer
p7 = foot_pt(FOOT_END, FOOT_V_BOT, -1)                                    # left bottom-outer
p6 = foot_pt(math.sqrt(R_BORE ** 2 - FOOT_V_BOT ** 2), FOOT_V_BOT, -1)    # left bottom-inner
p2, p3, p4, p5 = [(-p[0], p[1]) for p in (p1, p8, p7, p6)]               # mirrored right side
apex = (0.0, OUT_CZ + R_OUT)
bore_top = (0.0, R_BORE)

# ---------------- main body: profile in XZ, extruded along Y ----------------
profile = (
    cq.Workplane("XZ")
    .moveTo(*p6)
    .lineTo(*p7)
    .lineTo(*p8)
    .lineTo(*p1)
    .threePointArc(apex, p2)
    .lineTo(*p3)
    .lineTo(*p4)
    .lineTo(*p5)
    .threePointArc(bore_top, p6)
    .close()
)
body = profile.extrude(DEPTH / 2.0, both=True)

# counterbore in the front face
cbore = (
    cq.Workplane("XZ", origin=(0, YF, 0))
    .circle(R_CBORE)
    .extrude(-CBORE_DEPTH)
)
body = body.cut(cbore)

# bolt holes, normal to the tilted feet
for side in (-1, 1):
    hx, hz = foot_pt(HOLE_U, 0.0, side)
    hole = (
        cq.Workplane("XY")
        .circle(HOLE_D / 2.0)
        .extrude(80.0, both=True)
        .rotate((0, 0, 0), (0, 1, 0), -side * THETA)
        .translate((hx, 0, hz))
    )
    body = body.cut(hole)


# ---------------- edge treatment ----------------
def edge_filter(fn):
    class _Sel(cq.Selector):
        def filter(self, objs):
            return [o for o in objs if fn(o)]
    return _Sel()


def is_end_edge(e, yv):
    """Straight edge of a foot end face lying in the face plane Y = yv."""
    a, b = e.startPoint(), e.endPoint()
    return (abs(a.y - yv) < 1e-4 and abs(b.y - yv) < 1e-4
            and min(abs(a.x), abs(b.x)) > FOOT_END * c - 5.0
            and abs(a.x - b.x) < 15.0 and abs(a.z - b.z) > 10.0)


body = body.edges(edge_filter(lambda e: is_end_edge(e, YF))).fillet(END_FILLET)
body = body.edges(edge_filter(lambda e: is_end_edge(e, YB))).chamfer(END_CHAMFER)


def is_bore_bottom_edge(e):
    """Straight edges along Y where the bore / counterbore meet the foot bottoms."""
    a, b = e.startPoint(), e.endPoint()
    pts = [a, b, e.Center()]
    return (abs(a.y - b.y) > 1.0
            and all(R_BORE - 2.5 < abs(p.x) < R_CBORE + 1.0 and p.z < 12.0 for p in pts))


body = body.edges(edge_filter(is_bore_bottom_edge)).fillet(BORE_FILLET)


def is_back_rim_edge(e):
    """Every edge of the back face except the ones bounding the big end chamfers."""
    a, b = e.startPoint(), e.endPoint()
    if abs(a.y - YB) > 1e-4 or abs(b.y - YB) > 1e-4:
        return False
    if min(abs(a.x), abs(b.x)) > FOOT_END * c - 8.0 and abs(a.z - b.z) > 10.0:
        return False
    return True


body = body.edges(edge_filter(is_back_rim_edge)).chamfer(EDGE_CHAMFER)

result = body
